"""Moulded cover / hood with three indicator holes.

A thin-walled shell, open at the bottom, elongated along X:
  * vertical side walls, a ruled chamfer and a narrow crown facet on each side
    running up to a flat crown whose height follows a smooth spline along X;
  * octagonal plan: the ends narrow through vertical corner faces;
  * the -X end leans out to a tip (vertical just above the floor) with a small
    overhanging lip at its corners and a snap latch at the bottom centre;
  * the +X end is a hood: its underside slopes back to a recessed end block
    carrying a rounded central bar, two gusset ribs, two shallow corner pads
    and two mounting tabs with countersunk holes and concave tips;
  * three through holes of increasing size in the crown, each with a shallow
    counterbore that follows the crown surface.
The outer body is the intersection of three helper solids (a ruled "roof"
loft across Y, an XZ end profile and an XY plan prism); the cavity is the same
construction offset inwards by the wall thickness.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
HW = 52.5          # half width (Y) of the side walls
T = 2.5            # wall thickness
Z_CREASE = 33.6    # height of the side-wall / chamfer crease
Y_CH = 33.7        # chamfer upper edge (constant |y| along the length)
DZ_CH = 4.3        # drop of the chamfer upper edge below the crown line
Y_TOP = 24.7       # half width of the flat crown
Z_LIP = 0.6        # -X corner lip underside above the crease (at the kink)
LIP_RISE = 2.2     # rise of the lip underside towards the -X tip

# plan octagon (vertical corner faces)
XN_D0 = -60.0                  # -X diagonal starts on the side wall
XN_K, YN_K = -76.0, 46.0       # kink of the -X diagonal (then 45 deg below the lip)
XN_TIP, YN_TIP = -100.0, 30.5  # -X tip corner
R_SIDE = 30.0                  # blend radius side wall -> -X corner face
XP_D0 = 59.0                   # +X diagonal starts on the side wall
XP_K, YP_K = 91.0, 35.0        # kink of the +X diagonal near the tip
XP_TIP, YP_TIP = 100.0, 26.0   # +X tip corner

# side profile (XZ)
XN_BOT = -78.5     # -X end face at the bottom (leans out to the tip above)
Z_KNEE = 7.3       # the -X end is vertical below this height
Z_TIP_N = 37.1     # crown height at the -X tip
XP_WALL = 68.0     # +X end wall under the hood
Z_HOOD = 29.4      # hood underside meets the end wall
Z_TIP_P = 52.4     # crown height at the +X tip
# crown line (x, z) along the centre of the top
CROWN = [(-125.0, 32.0), (-100.0, Z_TIP_N), (-73.0, 42.7), (-49.0, 49.0),
         (-20.0, 56.2), (10.0, 60.7), (35.0, 62.5), (60.0, 60.5),
         (82.0, 56.5), (100.0, Z_TIP_P), (125.0, 45.5)]

# holes in the top (x, diameter) with a shallow counterbore that follows the top
HOLES = [(-41.6, 21.4), (-5.3, 28.4), (36.8, 35.8)]
CB_D, CB_DEPTH = 1.8, 1.0

# helper-solid extents
BIG = 300.0
ZLOW = -20.0
ZHIGH = 150.0

Z_PEAK = max(z for (_, z) in CROWN)


def crown_z(z, k, dz):
    """Crown height scaled by k about the crease height, dropped by dz."""
    return Z_CREASE + k * (z - Z_CREASE) - dz


def crown_edge(y, k, dz):
    pts = [cq.Vector(x, y, crown_z(z, k, dz)) for (x, z) in CROWN]
    return cq.Edge.makeSpline(pts)


def station_wire(y, k, dz, line_z=None):
    """Closed wire in the plane Y=y: top = crown line scaled by k and dropped
    by dz (or a straight line at line_z), sides and bottom straight."""
    x0, x1 = CROWN[0][0], CROWN[-1][0]
    if line_z is None:
        top = crown_edge(y, k, dz)
        z0 = crown_z(CROWN[0][1], k, dz)
        z1 = crown_z(CROWN[-1][1], k, dz)
    else:
        top = cq.Edge.makeLine(cq.Vector(x0, y, line_z), cq.Vector(x1, y, line_z))
        z0 = z1 = line_z
    zl = ZLOW - 7.0   # keep the bounding faces of the helper solids apart
    e2 = cq.Edge.makeLine(cq.Vector(x1, y, z1), cq.Vector(x1, y, zl))
    e3 = cq.Edge.makeLine(cq.Vector(x1, y, zl), cq.Vector(x0, y, zl))
    e4 = cq.Edge.makeLine(cq.Vector(x0, y, zl), cq.Vector(x0, y, z0))
    return cq.Wire.assembleEdges([top, e2, e3, e4])


def roof(off=0.0):
    """Solid bounded above by the crown, the two crown facets and the two
    ruled side chamfers (a ruled loft across Y)."""
    hw = HW - off
    ych = Y_CH - 0.4 * off
    yt = Y_TOP
    zc = Z_CREASE + 0.3 * off
    # The outermost stations run flat past the side walls so that no face of
    # this helper solid coincides with a face of the plan prism.  The chamfer
    # upper edge drops below the crown in proportion to the crown height above
    # the crease (DZ_CH at the peak, almost nothing at the -X tip).
    kc = 1.0 - DZ_CH / (Z_PEAK - Z_CREASE)
    stations = [(-hw - 10.0, 1.0, None, zc), (-hw, 1.0, None, zc), (-ych, kc, off, None),
                (-yt, 1.0, off, None), (yt, 1.0, off, None), (ych, kc, off, None),
                (hw, 1.0, None, zc), (hw + 10.0, 1.0, None, zc)]
    wires = [station_wire(y, k, dz if dz is not None else 0.0, lz) for (y, k, dz, lz) in stations]
    solid = cq.Solid.makeLoft(wires, True)
    return cq.Workplane("XY").add(solid)


def ends(off=0.0):
    """XZ profile giving the leaning -X end (vertical just above the floor),
    the +X hood underside and the +X end wall, extruded across the width."""
    kn = (XN_BOT - XN_TIP) / (Z_TIP_N - Z_KNEE)   # dx/dz of the -X end (lean)
    kp = (XP_TIP - XP_WALL) / (Z_TIP_P - Z_HOOD)  # dx/dz of the hood underside
    pts = [(XN_BOT, ZLOW), (XN_BOT, Z_KNEE),
           (XN_BOT - kn * (ZHIGH - Z_KNEE), ZHIGH),
           (XP_WALL + kp * (ZHIGH - Z_HOOD), ZHIGH),
           (XP_WALL, Z_HOOD), (XP_WALL, ZLOW)]
    w = cq.Workplane("XZ").polyline(pts).close()
    if off:
        w = w.offset2D(-off, "intersection")
    return w.extrude(BIG / 2, both=True)


def rounded_outline(z0, pts, radii):
    """Closed planar outline at height z0 through pts; vertices listed in
    radii (index -> radius) are rounded with tangent arcs."""
    n = len(pts)
    segs = []  # per vertex: (entry point, arc mid or None, exit point)
    for i, v in enumerate(pts):
        r = radii.get(i, 0.0)
        if r <= 0.0:
            segs.append((v, None, v))
            continue
        p, q = pts[i - 1], pts[(i + 1) % n]
        d1 = (v[0] - p[0], v[1] - p[1])
        d2 = (q[0] - v[0], q[1] - v[1])
        l1, l2 = math.hypot(*d1), math.hypot(*d2)
        d1 = (d1[0] / l1, d1[1] / l1)
        d2 = (d2[0] / l2, d2[1] / l2)
        th = math.acos(max(-1.0, min(1.0, d1[0] * d2[0] + d1[1] * d2[1])))
        t = r * math.tan(th / 2)
        b = (d2[0] - d1[0], d2[1] - d1[1])
        lb = math.hypot(*b)
        b = (b[0] / lb, b[1] / lb)
        h = r * (1.0 / math.cos(th / 2) - 1.0)
        segs.append(((v[0] - d1[0] * t, v[1] - d1[1] * t),
                     (v[0] + b[0] * h, v[1] + b[1] * h),
                     (v[0] + d2[0] * t, v[1] + d2[1] * t)))
    w = cq.Workplane("XY").workplane(offset=z0).moveTo(*segs[0][2])
    for i in range(1, n + 1):
        a, m, e = segs[i % n]
        w = w.lineTo(*a)
        if m is not None:
            w = w.threePointArc(m, e)
    return w.close()


def plan(off=0.0):
    """Octagonal plan with vertical corner faces.  Below the crease the -X
    corners are cut back at 45 deg, above it the top overhangs them as a lip
    following the shallower plan diagonal."""
    sn = (YN_K - YN_TIP) / (XN_K - XN_TIP)      # -X diagonal slope (2nd seg)
    sp = (YP_K - YP_TIP) / (XP_TIP - XP_K)      # +X diagonal slope (2nd seg)
    xe_n, xe_p = XN_TIP - 40.0, XP_TIP + 20.0
    yn = YN_TIP - 40.0 * sn
    yp = max(YP_TIP - 20.0 * sp, 2.0)
    right = [(XN_D0, HW), (XP_D0, HW), (XP_K, YP_K), (xe_p, yp), (xe_p, -yp),
             (XP_K, -YP_K), (XP_D0, -HW), (XN_D0, -HW), (XN_K, -YN_K)]
    upper = right + [(xe_n, -yn), (xe_n, yn), (XN_K, YN_K)]
    s45 = YN_K - 10.0
    lower = right + [(XN_K - s45, -10.0), (xe_n, -10.0), (xe_n, 10.0),
                     (XN_K - s45, 10.0), (XN_K, YN_K)]

    def prism(pts, z0, z1):
        # soft transition from the side walls into the -X corner faces
        w = rounded_outline(z0, pts, {0: R_SIDE, 7: R_SIDE})
        if off:
            w = w.offset2D(-off, "intersection")
        return w.extrude(z1 - z0)

    # the lip underside rises slightly towards the -X tip
    z_a = Z_CREASE + Z_LIP + 0.3 * off
    z_b = z_a + LIP_RISE
    sl = (z_b - z_a) / (XN_K - XN_TIP)
    xa, xb = XN_K + 200.0, XN_TIP - 60.0
    above = (cq.Workplane("XZ")
             .polyline([(xa, z_a - sl * 200.0), (xb, z_a + sl * (XN_K - xb)),
                        (xb, ZHIGH + 20.0), (xa, ZHIGH + 20.0)]).close()
             .extrude(BIG / 2, both=True))
    full = prism(lower, ZLOW - 3.0, ZHIGH + 5.0)
    lip = prism(upper, ZLOW - 3.0, ZHIGH + 5.0).intersect(above)
    return full.union(lip)


def body(off=0.0):
    b = roof(off).intersect(ends(off)).intersect(plan(off))
    if off == 0.0:
        b = b.intersect(cq.Workplane("XY").box(BIG, BIG, ZHIGH - 10.0, centered=(True, True, False)))
    return b


outer = body(0.0)
inner = body(T)
shell = outer.cut(inner)

# holes through the top, each with a surface-following counterbore ring
skin = outer.cut(outer.translate((0, 0, -CB_DEPTH)))
for (hx, hd) in HOLES:
    shell = shell.cut(cq.Workplane("XY").workplane(offset=20.0).center(hx, 0)
                      .circle(hd / 2).extrude(80.0))
    ring = (cq.Workplane("XY").workplane(offset=20.0).center(hx, 0)
            .circle(hd / 2 + CB_D / 2).extrude(80.0)).intersect(skin)
    shell = shell.cut(ring)

# snap latch hanging below the -X end
LATCH_W, LATCH_H, LATCH_T = 22.0, 8.0, 2.2
X_LATCH = XN_BOT + 0.2          # inner face of the latch plate
latch = (cq.Workplane("XY").box(LATCH_T, LATCH_W, LATCH_H, centered=(False, True, False))
         .translate((X_LATCH - LATCH_T, 0, 0)))
hook = (cq.Workplane("XY").box(1.5, LATCH_W, 1.6, centered=(False, True, False))
        .translate((X_LATCH - LATCH_T - 1.5, 0, 0)))
shell = shell.union(latch).union(hook)


# ---------------- +X end block (under the hood) ----------------
X_MID = 86.5        # front face of the central block
Z_MID = 31.0        # top of the central block
R_MID = 7.0         # round on its top front edge (the "hinge bar" look)
R_MIDV = 3.0        # round on its vertical front edges
Y_PAD0, Y_PAD1 = 30.6, 47.7   # corner pads / tabs span in |y|
X_PAD = 71.5        # front face of the shallow corner pads
Z_PAD = 28.0        # top of the corner pads
R_PAD = 2.5
TAB_T = 4.2         # mounting tab thickness
X_TAB_O = 89.0      # tab tip at its outer corner
X_TAB_I = 93.0      # tab tip at its inner corner
TAB_ARC = 3.0       # depth of the concave end arc
TAB_HOLE = (84.0, 39.2)
TAB_HD, TAB_CSK = 3.5, 7.5
RIB_Y0, RIB_Y1 = 11.5, 23.2   # gusset ribs span in |y|
RIB_X0, RIB_Z0 = 89.0, 27.0   # lower front corner of a rib
RIB_X1 = 98.0                 # upper end of the rib free edge

xw = XP_WALL - 0.5  # overlap into the shell end wall

mid = (cq.Workplane("XY").box(X_MID - xw, 2 * Y_PAD0, Z_MID, centered=False)
       .translate((xw, -Y_PAD0, 0)))
mid = mid.edges("|Z and >X").fillet(R_MIDV)
mid = mid.edges("|Y and >X and >Z").fillet(R_MID)
end_parts = mid

KP_HOOD = (XP_TIP - XP_WALL) / (Z_TIP_P - Z_HOOD)   # dx/dz of the hood underside


def hood_z(x):
    """Height of the hood underside at x."""
    return Z_HOOD + (x - XP_WALL) / KP_HOOD


for sgn in (1, -1):
    y0, y1 = sorted((sgn * (Y_PAD0 - 0.5), sgn * Y_PAD1))
    pad = (cq.Workplane("XY").box(X_PAD - xw, y1 - y0, Z_PAD, centered=False)
           .translate((xw, y0, 0)))
    pad = pad.edges("|Y and >X and >Z").fillet(R_PAD)
    # mounting tab with a concave end and a countersunk hole
    yc = sgn * (Y_PAD0 + Y_PAD1) / 2
    hw_t = (Y_PAD1 - Y_PAD0) / 2
    y_in, y_out = sgn * Y_PAD0, sgn * Y_PAD1
    x_mid = (X_TAB_O + X_TAB_I) / 2 - TAB_ARC
    tab = (cq.Workplane("XY")
           .moveTo(xw, y_out).lineTo(X_TAB_O, y_out)
           .threePointArc((x_mid, yc), (X_TAB_I, y_in))
           .lineTo(xw, y_in).close()
           .extrude(TAB_T))
    part_ = pad.union(tab)
    cone = cq.Solid.makeCone(TAB_CSK / 2, 0.0, TAB_CSK / 2,
                             pnt=cq.Vector(TAB_HOLE[0], sgn * TAB_HOLE[1], TAB_T),
                             dir=cq.Vector(0, 0, -1))
    hole = cq.Workplane("XY").add(cone).union(
        cq.Workplane("XY").center(TAB_HOLE[0], sgn * TAB_HOLE[1])
        .circle(TAB_HD / 2).extrude(TAB_T))
    part_ = part_.cut(hole)
    end_parts = end_parts.union(part_)

# gusset ribs between the central block and the hood underside
for sgn in (1, -1):
    y0, y1 = sorted((sgn * RIB_Y0, sgn * RIB_Y1))
    p_a = (xw, RIB_Z0)
    p_b = (RIB_X0, RIB_Z0)
    p_c = (RIB_X1, hood_z(RIB_X1) + 1.0)
    mx, mz = (p_b[0] + p_c[0]) / 2, (p_b[1] + p_c[1]) / 2
    rib = (cq.Workplane("XZ").workplane(offset=-y1)
           .moveTo(*p_a).lineTo(*p_b)
           .threePointArc((mx - 4.0, mz + 1.5), p_c)
           .lineTo(xw, hood_z(xw) + 1.0).close()
           .extrude(y1 - y0))
    end_parts = end_parts.union(rib)

result = shell.union(end_parts)
